import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 75.0          # plate width  (X)
D = 94.0          # plate depth  (Y)
T = 6.2           # plate thickness (plate top at Z=0)

XS = 19.65        # x of the right piece's left edge (= box left face)
YS = XS           # y of the left piece's front edge

# back-left step
STEP_Y = 82.5     # back edge of the left portion
STEP_X0 = 12.2    # start of the 45 deg step
STEP_X1 = 20.0    # x of the short vertical step at the back
BACK_R = 5.4      # plan radius of the back-right corner
STEP_R = 1.6      # radii at the step

# keyhole slot running at 45 deg toward the front-left
SLOT_R = 13.3
SLOT_BCH = 1.0   # bottom chamfer around the round end
SLOT_CX = 46.7
SLOT_CY = SLOT_CX + SLOT_R * math.sqrt(2)   # lower edge passes through (XS, XS)

# hook / latch at the slot entrance (left piece)
Q2 = (6.1, 35.3)  # bump tip
Q3 = (3.6, 32.0)
Q4 = (15.6, YS)
_k = ((Q2[1] - Q2[0]) - (SLOT_CY - SLOT_CX + SLOT_R * math.sqrt(2))) / (3.77 + 4.3)
Q1 = (Q2[0] + 3.77 * _k, Q2[1] - 4.3 * _k)   # where the hook meets the slot edge
HOOK_R = 2.2
BUMP_R = 1.0
TIP_R = 1.2
Q1_R = 1.5

# edge breaks on the plate top
BEV_W = 1.4       # back / right bevel: width on the top face
BEV_H = 3.3       # back / right bevel: height on the side faces
CH_SMALL = 0.45   # remaining top edges

# box hanging under the plate
BX0, BX1 = XS, 69.2
BY0, BY1 = XS, 39.2
BH = 24.8
BOX_R = 2.3
BOX_BOT_R = 0.0   # bottom edges of the box are left sharp
BOSS_R = 8.3       # round boss around the cross hole (shows at the box corners)
NOTCH_C = 10.0    # depth of the 45 deg relief of the box corner under the slot

# counterbored plate holes (with printed bridging layers)
HOLE_D = 3.5
CB_D = 7.6
CB_H = 3.9
CB_CH = 0.35
BRIDGE = 4.1
LAYER = 0.3
HOLES = [(26.9, 84.6), (65.5, 84.5), (7.3, 64.1), (65.5, 46.1), (45.8, 7.0)]

# underside strips and pads
STRIP_H = 1.1
PAD_H = 2.55
PAD_R = 1.2
FS_X0, FS_X1 = 23.2, 70.8    # front strip
FS_Y0, FS_Y1 = 3.6, 10.8
FS_PAD = 7.6
LS_X0, LS_X1 = 3.2, 11.1    # left strip
LS_Y0 = 48.6
LS_BEV = 2.4

# cross hole through the box (along X) with teardrop countersink
XH_D = 3.8
XH_CB_D = 7.4
XH_CB_H = 1.5
LENS_R = 6.4
LENS_TIP_TOP = 7.6
LENS_TIP_BOT = LENS_R * math.sqrt(2)
LENS_DEPTH = 13.0
XH_DY = 1.1
XH_DZ = 0.0


def plate_outline():
    s2 = math.sqrt(2) / 2
    t1 = (SLOT_CX - SLOT_R * s2, SLOT_CY + SLOT_R * s2)
    tm = (SLOT_CX + SLOT_R * s2, SLOT_CY + SLOT_R * s2)
    t2 = (SLOT_CX + SLOT_R * s2, SLOT_CY - SLOT_R * s2)
    wp = (cq.Workplane("XY")
          .moveTo(XS, 0)
          .lineTo(W, 0)
          .lineTo(W, D)
          .lineTo(STEP_X1, D)
          .lineTo(STEP_X1, STEP_Y + (STEP_X1 - STEP_X0))
          .lineTo(STEP_X0, STEP_Y)
          .lineTo(0, STEP_Y)
          .lineTo(0, YS)
          .lineTo(*Q4)
          .lineTo(*Q3)
          .lineTo(*Q2)
          .lineTo(*Q1)
          .lineTo(*t1)
          .threePointArc(tm, t2)
          .lineTo(XS, XS)
          .close())
    return wp


def vertical_edges_near(shape, pts, tol=0.3):
    """Return vertical edges of shape that pass through the given XY points."""
    sel = []
    for e in shape.Edges():
        p0 = e.startPoint()
        p1 = e.endPoint()
        if abs(p0.x - p1.x) > 1e-4 or abs(p0.y - p1.y) > 1e-4:
            continue
        for (x, y) in pts:
            if abs(p0.x - x) < tol and abs(p0.y - y) < tol:
                sel.append(e)
                break
    return sel


def fillet_vertical(wp, pts, r):
    s = wp.val()
    edges = vertical_edges_near(s, pts)
    return cq.Workplane("XY").newObject([s.fillet(r, edges)])


# ---------------- plate ----------------
plate = plate_outline().extrude(-T)
plate = fillet_vertical(plate, [(W, D)], BACK_R)
plate = fillet_vertical(plate, [Q4], HOOK_R)
plate = fillet_vertical(plate, [Q2], TIP_R)
plate = fillet_vertical(plate, [Q3], BUMP_R)
plate = fillet_vertical(plate, [Q1], Q1_R)
plate = fillet_vertical(plate, [(STEP_X1, STEP_Y + STEP_X1 - STEP_X0),
                                (STEP_X0, STEP_Y)], STEP_R)

# small chamfer on the top edges (slot, hook, front, left and back-left step);
# the back / right edges get the bigger rounded bevel below instead
def on_back_or_right(e):
    c = e.Center()
    return (c.x > W - 6 and c.y > 1) or (c.y > D - 6 and c.x > STEP_X1 + 0.5)


_small = [e for e in plate.faces(">Z").edges().vals() if not on_back_or_right(e)]
plate = cq.Workplane("XY").newObject([plate.val().chamfer(CH_SMALL, None, _small)])

# steep rounded bevel along the back edge, back-right corner and right edge:
# circular profile tangent to the side face BEV_H below the top and meeting
# the top face BEV_W in from the edge
_rb = (BEV_W ** 2 + BEV_H ** 2) / (2 * BEV_W)       # profile radius
_a0 = math.atan2(BEV_H, BEV_W - _rb)
_am = (_a0 + math.pi) / 2
_mid = (_rb + _rb * math.cos(_am), -BEV_H + _rb * math.sin(_am))   # (u, z)


def bevel_profile(wp, edge, sgn):
    """2D cutter profile; local x = edge + sgn*u (u measured inward)."""
    def p(u, z):
        return (edge - sgn * u, z)
    return (wp.moveTo(*p(-1, -BEV_H)).lineTo(*p(-1, 1)).lineTo(*p(BEV_W, 1))
            .lineTo(*p(BEV_W, 0)).threePointArc(p(*_mid), p(0, -BEV_H)).close())


_ccx, _ccy = W - BACK_R, D - BACK_R
_right = bevel_profile(cq.Workplane("XZ", origin=(0, _ccy, 0)), W, 1).extrude(_ccy + 1)
_back = bevel_profile(cq.Workplane("YZ", origin=(STEP_X1 - 1, 0, 0)), D, 1) \
    .extrude(_ccx - STEP_X1 + 1)
_corner = bevel_profile(cq.Workplane("XZ", origin=(0, _ccy, 0)), W, 1) \
    .revolve(90, (_ccx, 0, 0), (_ccx, 1, 0))
plate = plate.cut(_right).cut(_back).cut(_corner)

# chamfer on the bottom edge of the slot's round end (conical cutter that
# fades out along the straight slot sides)
_eps = 0.05
_cone = cq.Solid.makeCone(SLOT_R + SLOT_BCH + _eps, SLOT_R - 0.01, SLOT_BCH + _eps,
                          cq.Vector(SLOT_CX, SLOT_CY, -T - _eps), cq.Vector(0, 0, 1))
plate = plate.cut(cq.Workplane("XY").newObject([_cone]))

# ---------------- underside strips with pads ----------------
def block(x0, x1, y0, y1, h):
    return (cq.Workplane("XY").workplane(offset=-T)
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0).extrude(-h))


def pad(x0, x1, y0, y1, h, r):
    b = block(x0, x1, y0, y1, h)
    return b.edges("|Z").fillet(r)


# front strip (along X) with a pad at each end
strips = (block(FS_X0, FS_X1, FS_Y0, FS_Y1, STRIP_H)
          .union(pad(FS_X0, FS_X0 + FS_PAD, FS_Y0, FS_Y1, PAD_H, PAD_R))
          .union(pad(FS_X1 - FS_PAD, FS_X1, FS_Y0, FS_Y1, PAD_H, PAD_R)))
# left strip (along Y): front end bevelled parallel to the slot, pad at the back
left_strip = (cq.Workplane("XY").workplane(offset=-T)
              .polyline([(LS_X0, LS_Y0), (LS_X0 + LS_BEV, LS_Y0),
                         (LS_X1, LS_Y0 + (LS_X1 - LS_X0 - LS_BEV)),
                         (LS_X1, STEP_Y), (LS_X0, STEP_Y)])
              .close().extrude(-STRIP_H))
strips = (strips.union(left_strip)
          .union(pad(LS_X0, LS_X1, STEP_Y - 6.2, STEP_Y, PAD_H, PAD_R)))
# keep everything inside the plate outline
footprint = plate_outline().extrude(-(T + PAD_H + 1))
strips = strips.intersect(footprint)

# ---------------- box ----------------
box = (cq.Workplane("XY").workplane(offset=-T)
       .center((BX0 + BX1) / 2, (BY0 + BY1) / 2)
       .rect(BX1 - BX0, BY1 - BY0).extrude(-BH))
box = box.edges("|Z").fillet(BOX_R)
if BOX_BOT_R > 0:
    box = box.faces("<Z").edges().fillet(BOX_BOT_R)
# cylindrical boss around the cross-hole axis running the length of the box;
# it fills the rounded vertical corners locally
_zc = -T - BH / 2 - XH_DZ
_yc = (BY0 + BY1) / 2 + XH_DY
boss = (cq.Workplane("YZ").workplane(offset=BX0).center(_yc, _zc)
        .circle(BOSS_R).extrude(BX1 - BX0))
box = box.union(boss)

part = plate.union(box).union(strips)

# 45 deg relief of the box corner that sits under the slot
e = 1.0
tri = (cq.Workplane("XY").workplane(offset=-T - NOTCH_C - e)
       .polyline([(BX0 - e, BY1 + e), (BX0 - e, BX0 - e), (BY1 + e, BY1 + e)])
       .close().extrude(NOTCH_C + e + T + 1))
L = 200.0
h1 = (cq.Solid.makeBox(L, L, L, cq.Vector(-L / 2, -L / 2, 0))
      .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -45)
      .translate(cq.Vector(BX0, 0, -T - NOTCH_C)))
h2 = (cq.Solid.makeBox(L, L, L, cq.Vector(-L / 2, -L / 2, 0))
      .rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -45)
      .translate(cq.Vector(0, BY1, -T - NOTCH_C)))
relief = tri.intersect(cq.Workplane("XY").newObject([h1])).union(
    tri.intersect(cq.Workplane("XY").newObject([h2])))
part = part.cut(relief)

# ---------------- counterbored holes ----------------
def hole_cutter(hx, hy):
    """Counterbore + two printed bridging layers (slot, then square) + hole."""
    cb = (cq.Workplane("XY").workplane(offset=1).center(hx, hy)
          .circle(CB_D / 2).extrude(-(CB_H + 1)))
    br1 = (cq.Workplane("XY").workplane(offset=-CB_H + 0.01).center(hx, hy)
           .rect(BRIDGE, CB_D).extrude(-LAYER - 0.01))
    br1 = br1.intersect(cq.Workplane("XY").center(hx, hy)
                        .circle(CB_D / 2).extrude(-T))
    br2 = (cq.Workplane("XY").workplane(offset=-CB_H - LAYER + 0.01)
           .center(hx, hy).rect(BRIDGE, BRIDGE).extrude(-LAYER - 0.01))
    th = (cq.Workplane("XY").center(hx, hy).circle(HOLE_D / 2)
          .extrude(-(T + PAD_H + 2)))
    return cb.union(br1).union(br2).union(th)


for (hx, hy) in HOLES:
    part = part.cut(hole_cutter(hx, hy))

# small edge break on the counterbore rims
_rims = []
for _e in part.edges().vals():
    if _e.geomType() == "CIRCLE" and abs(_e.Center().z) < 1e-3 \
            and abs(_e.radius() - CB_D / 2) < 1e-3:
        _rims.append(_e)
part = cq.Workplane("XY").newObject([part.val().chamfer(CB_CH, None, _rims)])

# ---------------- cross hole through the box ----------------
zc = -T - BH / 2 - XH_DZ
yc = (BY0 + BY1) / 2 + XH_DY
xh = (cq.Workplane("YZ").workplane(offset=BX0 - 5).center(yc, zc)
      .circle(XH_D / 2).extrude(BX1 - BX0 + 10))
part = part.cut(xh)

# teardrop-shaped pocket on the +X face: 45 deg point at the bottom (print
# overhang) and a blunter point at the top
r = LENS_R


def tangent_pt(d):
    c = r / d
    return r * math.sqrt(1 - c * c), r * c


ty1, tz1 = tangent_pt(LENS_TIP_TOP)
ty2, tz2 = tangent_pt(LENS_TIP_BOT)
lens = (cq.Workplane("YZ").workplane(offset=BX1 + 0.5).center(yc, zc)
        .moveTo(0, LENS_TIP_TOP)
        .lineTo(ty1, tz1)
        .threePointArc((r, 0), (ty2, -tz2))
        .lineTo(0, -LENS_TIP_BOT)
        .lineTo(-ty2, -tz2)
        .threePointArc((-r, 0), (-ty1, tz1))
        .close()
        .extrude(-(LENS_DEPTH + 0.5)))
part = part.cut(lens)
cbx = (cq.Workplane("YZ").workplane(offset=BX1 - LENS_DEPTH + 0.01).center(yc, zc)
       .circle(XH_CB_D / 2).extrude(-XH_CB_H))
part = part.cut(cbx)

result = part
